import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# origin: horn axis at X=0,Y=0 ; Z=0 at underside of servo case
BOX_X0, BOX_X1 = -32.5, 10.5      # servo case X extent
BOX_HW = 13.0                     # servo case half width (Y)
BOX_H = 38.6                      # servo case height
SEAM_Z = (23.4, 31.2)             # horizontal seams on case
CASE_CH = 1.5                     # vertical edge chamfer on case
SEAM_INSET = 0.5                  # inset of the case section above the upper seam

UB_X0 = -34.9                     # upper bracket -X face
UB_XP = 15.0                      # upper bracket +X recessed panel face
UB_XT = 21.5                      # upper bracket +X lip face
UB_HW = 15.6                      # upper bracket half width (Y)
UB_Z0, UB_Z1 = 38.6, 64.3         # upper bracket bottom / top
LIP_T = 3.0                       # top lip thickness on +X side
UB_CH = 1.8                       # top edge chamfer
RIB_T = 1.8                       # ribs under the +X lip
CORNER_C = 2.2                    # vertical corner chamfer at +X/±Y

WING_HW = 16.6                    # wing half width (X)
WING_Y0 = 15.35                   # wing inner end |Y|
WING_BEV = 2.35                   # bevel at the inner end
WING_Y1 = 59.3                    # wing tip |Y|
WING_Z0, WING_Z1 = 62.2, 67.5     # wing bottom / top
WING_R = 3.0                      # tip corner radius
SLOT_Y0, SLOT_Y1 = 20.0, 53.0     # slot extent |Y|
SLOT_W = 5.3
CHAN_HW = 6.9                     # shallow channel half width on wing top
CHAN_D = 0.5
CHAN_FLARE = 4.9
NOTCH_X, NOTCH_W, NOTCH_H = 12.5, 2.2, 2.6
POCKET_HW, POCKET_D = 11.4, 2.2     # pocket on wing underside
TIP_BAR = 2.5                     # cross bar left at the wing tip
SLOT_RIM = 1.2                    # rim left around the slot
SLOT_RIM_H = 0.4                  # rim height below the pocket floor

WEB_X, WEB_T = 10.3, 2.2          # gusset webs
WEB_Y1 = 52.8                     # web reach along wing underside
WEB_ZB = 39.5                     # web bottom at body

PL_X0, PL_X1 = -30.4, 1.1         # side plate X extent
PL_Z0, PL_Z1 = 5.6, 57.0          # side plate Z extent
PL_Y0, PL_T = 15.8, 2.2           # side plate inner |Y| and thickness
PL_R = 3.0
PL_SLOT_CLR = 0.5                 # clearance of plate slot around the web
PL_FL_T = 2.0                     # flange thickness (bent back to the case)
PL_BEND_R = 2.0                   # outer bend radius plate/flange
HOLE_X = (-25.8, -3.6)
HOLE_Z = (10.1, 20.9, 41.4, 52.6)
HOLE_D, CSK_D = 2.1, 5.0
WIN_OX0, WIN_OX1, WIN_OZ0, WIN_OZ1 = -19.7, -6.4, 27.4, 35.1   # plate window
WIN_X0, WIN_X1, WIN_Z0, WIN_Z1 = -17.3, -7.2, 27.8, 34.5       # case pocket
THRU_X0, THRU_X1 = -14.0, -7.7                                 # through passage

BOLT_PTS = [(-29.45, 10.1), (-29.45, -10.1), (7.6, -10.1), (7.6, 10.1)]
BOLT_D, BOLT_H, BOLT_HOLE = 6.4, 2.8, 3.6

HORN_R = 10.7                     # horn recess radius
HORN_D = 1.5
HORN_FLARE = 0.7                  # radial flare per 3 mm of height
HORN_HUB_R = 9.0
HORN_NUT_R = 3.6
HORN_BOLT_R = 1.9
HORN_BOLT_TOP = 68.6

BOT_PLATE_R = 9.2
BOT_BOSS_R = 3.5
BOT_SHAFT_R = 2.15
BOT_SCREWS = [(-30.0, 10.8), (-30.0, -10.8), (8.0, 10.8), (8.0, -10.8)]
BOT_SMALL_HOLES = [(-7.4, 10.5), (-7.4, -10.5)]
XFACE_HOLES = [(-6.5, 9.1), (6.5, 9.1), (-6.5, 19.6), (6.5, 19.6)]   # (Y, Z) on -X face
XFACE_NOTCH_Y = 8.5               # small notches in -X face bottom edge of bracket


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def compound(wps):
    tool = wps[0]
    for w in wps[1:]:
        tool = tool.union(w)
    return tool


# ---------------- servo case ----------------
case = box(BOX_X0, BOX_X1, -BOX_HW, BOX_HW, 0, SEAM_Z[1]).edges("|Z").chamfer(CASE_CH)
# middle shell section sits slightly inset above the upper seam
case_top = (box(BOX_X0 + SEAM_INSET, BOX_X1 - SEAM_INSET, -BOX_HW + SEAM_INSET,
                BOX_HW - SEAM_INSET, SEAM_Z[1] - 0.1, BOX_H)
            .edges("|Z").chamfer(CASE_CH - SEAM_INSET / 2))
case = case.union(case_top)

cut_list = []
zs = SEAM_Z[0]
ring = box(BOX_X0 - 1, BOX_X1 + 1, -BOX_HW - 1, BOX_HW + 1, zs - 0.2, zs + 0.2)
inner = box(BOX_X0 + 0.4, BOX_X1 - 0.4, -BOX_HW + 0.4, BOX_HW - 0.4, zs - 0.3, zs + 0.3)
cut_list.append(ring.cut(inner))
# small square recess on +X face
cut_list.append(box(BOX_X1 - 0.8, BOX_X1 + 1, -3.4, 3.4, 27.6, 34.2))
case = case.cut(compound(cut_list))

# ---------------- upper bracket ----------------
ub = (cq.Workplane("XZ", origin=(0, UB_HW, 0))
      .polyline([(UB_X0, UB_Z0), (UB_XP, UB_Z0), (UB_XP, UB_Z1 - LIP_T),
                 (UB_XT, UB_Z1 - LIP_T), (UB_XT, UB_Z1), (UB_X0, UB_Z1)]).close()
      .extrude(2 * UB_HW))
ub = ub.faces(">Z").edges().chamfer(UB_CH)
ub = ub.edges("|Z").edges("<X").chamfer(1.2)
# triangular ribs under the +X lip
for ry in (-UB_HW, -RIB_T / 2, UB_HW - RIB_T):
    rib = (cq.Workplane("XZ", origin=(0, ry + RIB_T, 0))
           .polyline([(UB_XP - 0.5, UB_Z0 + 0.7), (UB_XP, UB_Z0 + 0.7),
                      (UB_XT, UB_Z1 - LIP_T + 0.01), (UB_XT, UB_Z1 - LIP_T + 0.5),
                      (UB_XP - 0.5, UB_Z1 - LIP_T + 0.5)]).close()
           .extrude(RIB_T))
    ub = ub.union(rib)

# vertical corner chamfers at the +X/±Y corners (they fade out down the sloped ribs)
for s in (-1, 1):
    cc = (cq.Workplane("XY", origin=(0, 0, UB_Z0 - 1))
          .polyline([(UB_XT + 1, s * (UB_HW - CORNER_C - 1)), (UB_XT - CORNER_C - 1, s * (UB_HW + 1)),
                     (UB_XT + 1, s * (UB_HW + 1))]).close()
          .extrude(UB_Z1 - UB_Z0 + 2))
    ub = ub.cut(cc)
# small split notch in the +X lip at Y=0
ub = ub.cut(box(UB_XT - 0.8, UB_XT + 1, -0.5, 0.5, UB_Z1 - LIP_T - 1, UB_Z1 + 1))
# two small notches in the bottom edge of the -X face
for ny in (-XFACE_NOTCH_Y, XFACE_NOTCH_Y):
    ub = ub.cut(cq.Workplane("YZ", origin=(UB_X0 - 0.5, ny, UB_Z0))
                .slot2D(7.0, 1.8, 90).extrude(2.0))

body = case.union(ub)


# ---------------- wings ----------------
def wing(sign):
    w = box(-WING_HW, WING_HW, WING_Y0, WING_Y1, WING_Z0, WING_Z1)
    # 45 deg bevel at the inner end, running down onto the bracket top
    bev = (cq.Workplane("YZ", origin=(-WING_HW, 0, 0))
           .polyline([(WING_Y0 - WING_BEV, UB_Z1), (WING_Y0 + 0.01, UB_Z1 + WING_BEV),
                      (WING_Y0 + 0.01, WING_Z0 + 0.1), (WING_Y0 - WING_BEV, WING_Z0 + 0.1)]).close()
           .extrude(2 * WING_HW))
    w = w.union(bev)
    w = w.edges("|Z").edges(">Y").fillet(WING_R)
    cuts = []
    # slot
    cuts.append(cq.Workplane("XY", origin=(0, (SLOT_Y0 + SLOT_Y1) / 2, WING_Z0 - 1))
                .slot2D(SLOT_Y1 - SLOT_Y0, SLOT_W, 90).extrude(WING_Z1 - WING_Z0 + 2))
    # shallow channel on top, flaring at the inner end
    ch = (cq.Workplane("XY", origin=(0, 0, WING_Z1 - CHAN_D))
          .polyline([(-CHAN_HW, WING_Y1 + 2), (CHAN_HW, WING_Y1 + 2),
                     (CHAN_HW, UB_HW + 2.9), (CHAN_HW + CHAN_FLARE, UB_HW),
                     (CHAN_HW + CHAN_FLARE, UB_HW - 3), (-CHAN_HW - CHAN_FLARE, UB_HW - 3),
                     (-CHAN_HW - CHAN_FLARE, UB_HW), (-CHAN_HW, UB_HW + 2.9)]).close()
          .extrude(2))
    cuts.append(ch)
    # underside grooves (visible as notches at the tip)
    for nx in (-NOTCH_X, NOTCH_X):
        cuts.append(box(nx - NOTCH_W / 2, nx + NOTCH_W / 2, UB_HW + 0.5, WING_Y1 + 1,
                        WING_Z0 - 1, WING_Z0 + NOTCH_H))
    # underside pocket, leaving a tip cross bar and a rim around the slot
    pk = box(-POCKET_HW, POCKET_HW, UB_HW, WING_Y1 - TIP_BAR, WING_Z0 - 1, WING_Z0 + POCKET_D)
    rim = (cq.Workplane("XY", origin=(0, (SLOT_Y0 + SLOT_Y1) / 2,
                                      WING_Z0 + POCKET_D - SLOT_RIM_H))
           .slot2D(SLOT_Y1 - SLOT_Y0 + 2 * SLOT_RIM, SLOT_W + 2 * SLOT_RIM, 90)
           .extrude(SLOT_RIM_H + 1))
    cuts.append(pk.cut(rim))
    w = w.cut(compound(cuts))
    # gusset webs
    for wx in (-WEB_X, WEB_X):
        web = (cq.Workplane("YZ", origin=(wx - WEB_T / 2, 0, 0))
               .polyline([(UB_HW - 0.5, WING_Z0 + POCKET_D + 0.3),
                          (WING_Y1 - TIP_BAR + 0.3, WING_Z0 + POCKET_D + 0.3),
                          (WING_Y1 - TIP_BAR + 0.3, WING_Z0), (WEB_Y1, WING_Z0),
                          (UB_HW - 0.5, WEB_ZB)]).close()
               .extrude(WEB_T))
        w = w.union(web)
    if sign < 0:
        w = w.mirror("XZ")
    return w


body = body.union(wing(1)).union(wing(-1))


# ---------------- side plates ----------------
def side_plate():
    # built for +Y side, mirrored for -Y
    y0, y1 = PL_Y0, PL_Y0 + PL_T
    sx0 = -WEB_X - WEB_T / 2 - PL_SLOT_CLR
    sx1 = -WEB_X + WEB_T / 2 + PL_SLOT_CLR
    zs = WEB_ZB - 0.5
    ya, yb = BOX_HW - 1.0, y1 + 1.0
    # outline of the plate seen from the side (slot for the gusset web at the top)
    low = box(PL_X0, PL_X1, ya, yb, PL_Z0, zs + 1.0)
    low = low.edges("|Y").edges("<Z").edges("<X").fillet(PL_R)
    low = low.edges("|Y").edges("<Z").edges(">X").fillet(1.0)
    upl = box(PL_X0, sx0, ya, yb, zs, PL_Z1).edges("|Y").edges(">Z").fillet(1.6)
    upr = box(sx1, PL_X1, ya, yb, zs, PL_Z1).edges("|Y").edges(">Z").fillet(1.6)
    outline = low.union(upl).union(upr)
    # L-shaped sheet section: plate plus flange bent back to the case at +X edge
    sec = (cq.Workplane("XY", origin=(0, 0, PL_Z0 - 1))
           .polyline([(PL_X0, y0), (PL_X0, y1), (PL_X1, y1), (PL_X1, BOX_HW - 0.5),
                      (PL_X1 - PL_FL_T, BOX_HW - 0.5), (PL_X1 - PL_FL_T, y0)]).close()
           .extrude(PL_Z1 - PL_Z0 + 2))
    sec = sec.edges("|Z").edges(">X").edges(">Y").fillet(PL_BEND_R)
    pl = sec.intersect(outline)
    cuts = []
    for hx in HOLE_X:
        for hz in HOLE_Z:
            cuts.append(cq.Workplane("XZ", origin=(hx, y1 + 0.5, hz))
                        .circle(HOLE_D / 2).extrude(PL_T + 1.0))
            cs = cq.Solid.makeCone(CSK_D / 2, HOLE_D / 2, (CSK_D - HOLE_D) / 2,
                                   cq.Vector(hx, y1, hz), cq.Vector(0, -1, 0))
            cuts.append(cq.Workplane("XY").add(cs))
            cuts.append(cq.Workplane("XZ", origin=(hx, y1 + 1.0, hz))
                        .circle(CSK_D / 2).extrude(1.0))
    # window in the plate
    cuts.append(box(WIN_OX0, WIN_OX1, y0 - 0.5, y1 + 0.5, WIN_OZ0, WIN_OZ1))
    pl = pl.cut(compound(cuts))
    return pl


sp = side_plate()
body = body.union(sp).union(sp.mirror("XZ"))

# case pocket behind the windows and a through passage
wcuts = [box(WIN_X0, WIN_X1, BOX_HW - 4.0, BOX_HW + 1.0, WIN_Z0, WIN_Z1),
         box(WIN_X0, WIN_X1, -BOX_HW - 1.0, -BOX_HW + 4.0, WIN_Z0, WIN_Z1),
         box(THRU_X0, THRU_X1, -BOX_HW - 2.0, BOX_HW + 2.0, WIN_Z0, WIN_Z1)]
body = body.cut(compound(wcuts))

# ---------------- top details ----------------
hub = (cq.Workplane("XY", origin=(0, 0, UB_Z1 - HORN_D)).polygon(10, 2 * HORN_HUB_R)
       .extrude(0.8))
nut = (cq.Workplane("XY", origin=(0, 0, UB_Z1 - HORN_D + 0.8)).polygon(8, 2 * HORN_NUT_R)
       .extrude(HORN_D + 0.5).faces("<Z").edges().chamfer(0.6))
hb = (cq.Workplane("XY", origin=(0, 0, UB_Z1 + 0.3)).circle(HORN_BOLT_R)
      .extrude(HORN_BOLT_TOP - UB_Z1 - 0.3)
      .faces(">Z").workplane().polygon(6, 2.2).cutBlind(-1.2))


def bolt_head(bx, by):
    return (cq.Workplane("XY", origin=(bx, by, UB_Z1 - 0.2)).circle(BOLT_D / 2)
            .extrude(0.8)
            .faces(">Z").workplane().circle(BOLT_D / 2 - 0.3).extrude(BOLT_H - 0.6)
            .faces(">Z").edges().chamfer(0.5)
            .faces(">Z").workplane().circle(BOLT_HOLE / 2).cutBlind(-1.6))


for (bx, by) in BOLT_PTS[:-1]:
    body = body.union(bolt_head(bx, by))

# horn recess (its flared mouth also bites into the neighbouring bolt heads)
horn_cut = cq.Workplane("XY", origin=(0, 0, UB_Z1 - HORN_D)).circle(HORN_R).extrude(HORN_D)
horn_cone = cq.Solid.makeCone(HORN_R, HORN_R + HORN_FLARE * 2, 6.0,
                              cq.Vector(0, 0, UB_Z1), cq.Vector(0, 0, 1))
body = body.cut(horn_cut.union(cq.Workplane("XY").add(horn_cone)))
# the +Y bolt next to the horn is fitted after the recess and stays whole
body = body.union(bolt_head(*BOLT_PTS[-1]))
body = body.union(hub).union(nut).union(hb)

# ---------------- bottom details ----------------
bp = (cq.Workplane("XY", origin=(0, 0, -1.7)).polygon(10, 2 * BOT_PLATE_R).extrude(1.8)
      .faces("<Z").workplane().circle(BOT_PLATE_R - 2.2).cutBlind(-0.8))
bb = cq.Workplane("XY", origin=(0, 0, -3.8)).circle(BOT_BOSS_R).extrude(3.2)
bs = cq.Workplane("XY", origin=(0, 0, -6.2)).circle(BOT_SHAFT_R).extrude(2.5)
body = body.union(bp).union(bb).union(bs)

bcuts = []
for (bx, by) in BOT_SCREWS:
    bcuts.append(cq.Workplane("XY", origin=(bx, by, -0.1)).circle(1.2).extrude(0.8))
for (bx, by) in BOT_SMALL_HOLES:
    bcuts.append(cq.Workplane("XY", origin=(bx, by, -0.1)).circle(0.7).extrude(2.0))
# small holes on -X face of case
for (hy, hz) in XFACE_HOLES:
    bcuts.append(cq.Workplane("YZ", origin=(BOX_X0 - 0.1, hy, hz)).circle(0.8).extrude(2))
body = body.cut(compound(bcuts))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
